"""Three-way branching manifold on a three-lobe bolting flange.

A round trunk rises from a flat, three-lobed flange and splits into three tubes
(120 degrees apart) that curve outwards and end, leaning slightly inwards, in short
spigots.  The part is hollow: a large bore in the flange branches into the three tubes.

Construction
  * every branch is a circle swept along a spline centre line, its radius following a
    smooth law (trunk radius at the flange -> tube radius at the top); the inner passage
    is the same sweep with smaller radii
  * inside the 120 degree sector around a branch, the union of the three branches is just
    that branch, so one sector (branch + spigot - passage + flange sector) is built with
    ordinary booleans and the three identical sectors are stitched along their borders
  * the crotches between neighbouring branches are blended with a fillet
"""
import math
import cadquery as cq
from OCP.gp import gp_Ax2, gp_Pnt, gp_Dir, gp_Circ, gp_Pnt2d
from OCP.BRepOffsetAPI import BRepOffsetAPI_MakePipeShell
from OCP.Law import Law_Interpol
from OCP.TColgp import TColgp_Array1OfPnt2d
from OCP.BRepBuilderAPI import (BRepBuilderAPI_MakeEdge, BRepBuilderAPI_MakeWire,
                                BRepBuilderAPI_Sewing, BRepBuilderAPI_MakeSolid)
from OCP.BRepFilletAPI import BRepFilletAPI_MakeFillet
from OCP.ShapeUpgrade import ShapeUpgrade_UnifySameDomain
from OCP.TopExp import TopExp
from OCP.TopTools import TopTools_IndexedDataMapOfShapeListOfShape
from OCP.TopAbs import TopAbs_EDGE, TopAbs_FACE
from OCP.TopoDS import TopoDS
from OCP.BRepLib import BRepLib

# ---------------- driving dimensions (mm) ----------------
# flange (occupies z = -FLANGE_T .. 0)
FLANGE_T = 7.8
BOLT_R = 39.5           # radius of the bolt-hole / lobe centres
LOBE_R = 13.75          # outer radius of each lobe
HOLE_D = 12.0           # bolt hole diameter
SIDE_MIN = 30.0         # closest approach of the concave flange sides to the axis
LOBE_ANGLES = (30.0, 150.0, 270.0)

# trunk and branches
TRUNK_R = 26.45         # outer radius of the trunk where it meets the flange
TRUNK_BORE_R = 20.4     # bore radius at the bottom (through the flange)
BRANCH_ANGLES = (90.0, 210.0, 330.0)
# branch centre line in its own vertical plane: (radial offset, height)
PATH = [(0.0, 0.0), (0.58, 8.0), (3.0, 24.0), (9.66, 40.0), (22.04, 55.0), (31.01, 68.0),
        (39.22, 80.0), (42.44, 92.0), (43.8, 103.0)]
END_SLOPE = -0.07       # tube ends lean slightly inwards (dr/dz of the centre line at the top)
# outer radius of the swept circle at every path point
RADII = [TRUNK_R, 26.32, 25.53, 24.55, 18.44, 14.46, 13.8, 13.4, 13.2]
TUBE_R = RADII[-1]      # tube radius at the end (shoulder)
TUBE_BORE_R = 8.7       # bore of tube and spigot
SPIGOT_R = 10.8         # spigot outer radius
SPIGOT_H = 7.0          # spigot height above the shoulder
CROTCH_R = 11.0         # blend radius in the crotches between branches


# ---------------- branches ----------------
def inner_radius(r):
    # wall thins from the trunk to the tubes
    t = (TRUNK_R - r) / (TRUNK_R - TUBE_R)
    return TRUNK_BORE_R + (TUBE_BORE_R - TRUNK_BORE_R) * t


def branch_path(ang_deg):
    a = math.radians(ang_deg)
    u, z = cq.Vector(math.cos(a), math.sin(a), 0), cq.Vector(0, 0, 1)
    pts = [u * d + z * h for d, h in PATH]
    params = [0.0]
    for i in range(1, len(pts)):
        params.append(params[-1] + (pts[i] - pts[i - 1]).Length)
    e = cq.Edge.makeSpline(pts, tangents=[z, (u * END_SLOPE + z).normalized()],
                           parameters=params, scale=True)
    return e, params, u


def branch_solid(ang_deg, inner=False):
    """circle swept along the branch centre line, its radius following a smooth law"""
    e, params, u = branch_path(ang_deg)
    radii = [inner_radius(r) if inner else r for r in RADII]
    c0 = e.positionAt(params[0], mode="parameter")
    t0 = e.tangentAt(params[0], mode="parameter")
    circ = BRepBuilderAPI_MakeEdge(gp_Circ(gp_Ax2(gp_Pnt(*c0.toTuple()), gp_Dir(*t0.toTuple()),
                                                  gp_Dir(*u.toTuple())), radii[0])).Edge()
    profile = BRepBuilderAPI_MakeWire(circ).Wire()
    law_pts = TColgp_Array1OfPnt2d(1, len(radii))
    for i, (prm, r) in enumerate(zip(params, radii)):
        law_pts.SetValue(i + 1, gp_Pnt2d(prm, r / radii[0]))
    law = Law_Interpol()
    law.Set(law_pts, False)
    pipe = BRepOffsetAPI_MakePipeShell(cq.Wire.assembleEdges([e]).wrapped)
    pipe.SetMode(False)
    pipe.SetLaw(profile, law, False, False)
    pipe.Build()
    pipe.MakeSolid()
    return cq.Shape.cast(pipe.Shape())


def wedge(ang_deg, z0, z1=140.0, L=300.0):
    """120 degree sector prism centred on the branch direction"""
    pts = [(0.0, 0.0)]
    for da in (-60.0, -30.0, 0.0, 30.0, 60.0):
        a = math.radians(ang_deg + da)
        pts.append((L * math.cos(a), L * math.sin(a)))
    return cq.Workplane("XY").workplane(offset=z0).polyline(pts).close().extrude(z1 - z0)


def branch_piece(ang):
    e, params, u = branch_path(ang)
    c = e.positionAt(params[-1], mode="parameter")
    n = e.tangentAt(params[-1], mode="parameter")
    outer = cq.Workplane().add(branch_solid(ang))
    spigot = cq.Solid.makeCylinder(SPIGOT_R, SPIGOT_H + 0.5, c - n * 0.5, n)
    outer = outer.union(cq.Workplane().add(spigot))
    inner = cq.Workplane().add(branch_solid(ang, inner=True))
    bore = cq.Solid.makeCylinder(TUBE_BORE_R, SPIGOT_H + 6.0, c - n * 2.0, n)
    inner = inner.union(cq.Workplane().add(bore))
    return outer.cut(inner).intersect(wedge(ang, -1.0))


# ---------------- flange ----------------
def flange():
    u = BOLT_R * 0.5
    # concave side arcs tangent to neighbouring lobes, SIDE_MIN from the axis
    Dc = (BOLT_R ** 2 - (LOBE_R - SIDE_MIN) ** 2) / (2.0 * (u + LOBE_R - SIDE_MIN))
    Rc = Dc - SIDE_MIN
    sides = [a + 60.0 for a in LOBE_ANGLES]

    def tangent_pt(side_deg, lobe_deg):
        b, la = math.radians(side_deg), math.radians(lobe_deg)
        C = (Dc * math.cos(b), Dc * math.sin(b))
        L = (BOLT_R * math.cos(la), BOLT_R * math.sin(la))
        vx, vy = L[0] - C[0], L[1] - C[1]
        ln = math.hypot(vx, vy)
        return (C[0] + vx * Rc / ln, C[1] + vy * Rc / ln)

    wp = cq.Workplane("XY").workplane(offset=-FLANGE_T)
    start = tangent_pt(sides[2], LOBE_ANGLES[0] + 360.0)
    wp = wp.moveTo(*start)
    for i, la in enumerate(LOBE_ANGLES):
        a = math.radians(la)
        mid = ((BOLT_R + LOBE_R) * math.cos(a), (BOLT_R + LOBE_R) * math.sin(a))
        wp = wp.threePointArc(mid, tangent_pt(sides[i], la))
        b = math.radians(sides[i])
        cmid = (SIDE_MIN * math.cos(b), SIDE_MIN * math.sin(b))
        cend = start if i == 2 else tangent_pt(sides[i], LOBE_ANGLES[i + 1])
        wp = wp.threePointArc(cmid, cend)
    plate = wp.close().extrude(FLANGE_T)
    pts = [(BOLT_R * math.cos(math.radians(a)), BOLT_R * math.sin(math.radians(a))) for a in LOBE_ANGLES]
    cut = (cq.Workplane("XY").workplane(offset=-FLANGE_T - 1).pushPoints(pts)
           .circle(HOLE_D / 2).extrude(FLANGE_T + 2))
    cut = cut.union(cq.Workplane("XY").workplane(offset=-FLANGE_T - 1)
                    .circle(TRUNK_BORE_R).extrude(FLANGE_T + 1.0))
    return plate.cut(cut)


# ---------------- assemble: one 120 degree sector, patterned three times ----------------
a0 = BRANCH_ANGLES[0]
sector = branch_piece(a0).union(flange().intersect(wedge(a0, -FLANGE_T - 1.0)))

faces = []
for f in sector.val().Faces():
    if f.geomType() == "PLANE":
        n, c = f.normalAt(), f.Center()
        if abs(n.z) < 1e-6 and abs(n.dot(c)) < 1e-4:
            continue  # internal border face on a sector plane
    faces.append(f)

sew = BRepBuilderAPI_Sewing(1e-3)
for k in range(3):
    for f in faces:
        g = f if k == 0 else f.rotate(cq.Vector(0, 0, 0), cq.Vector(0, 0, 1), 120.0 * k)
        sew.Add(g.wrapped)
sew.Perform()
solid = BRepBuilderAPI_MakeSolid(TopoDS.Shell_s(sew.SewedShape())).Solid()
BRepLib.OrientClosedSolid_s(solid)
body = cq.Solid(solid)

# ---------------- crotch blends ----------------
# the outer creases between neighbouring branches lie on the sector planes (30/150/270 deg)
emap = TopTools_IndexedDataMapOfShapeListOfShape()
TopExp.MapShapesAndAncestors_s(body.wrapped, TopAbs_EDGE, TopAbs_FACE, emap)
crease = []
for i in range(1, emap.Extent() + 1):
    e = cq.Edge(emap.FindKey(i))
    fs = [cq.Face(f) for f in emap.FindFromIndex(i)]
    if len(fs) == 2 and all(f.geomType() == "BSPLINE" for f in fs) and e.geomType() == "BSPLINE":
        c = e.Center()
        ang = math.degrees(math.atan2(c.y, c.x)) % 360
        if min(abs(ang - a) for a in (30.0, 150.0, 270.0)) < 2:
            crease.append((math.hypot(c.x, c.y), e))
crease.sort(key=lambda t: -t[0])
for radius in (CROTCH_R, CROTCH_R + 1.0, CROTCH_R - 1.0, CROTCH_R - 2.0):
    mf = BRepFilletAPI_MakeFillet(body.wrapped)
    for _, e in crease[:3]:
        mf.Add(radius, e.wrapped)
    try:
        mf.Build()
        if mf.IsDone():
            blended = cq.Shape.cast(mf.Shape())
            if blended.isValid():
                body = blended
                break
    except Exception:
        pass

# merge coplanar / coaxial faces split by the sector stitching
unify = ShapeUpgrade_UnifySameDomain(body.wrapped, True, True, True)
unify.Build()
merged = cq.Shape.cast(unify.Shape())
if merged.isValid():
    body = merged

result = cq.Workplane("XY").add(body)
VIEW = {"azimuth": 45, "elevation": 26}
